import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 233.0          # plate length (front face y=0 -> back y=L)
W_BACK = 167.0     # plate width at the back (parallel section)
W_FRONT = 147.5    # plate width at the front face
TAPER_LEN = 100.0  # taper/straight corner position, measured from the front
BLEND = 4.0        # half length of the smooth blend between taper and side
T = 5.0            # plate thickness

H = 29.5           # wall height (from plate underside)
TW = 7.7           # wall thickness
NOTCH_BOT = 19.0   # half width of notch at the bottom (plate top)
NOTCH_TOP = 33.0   # half width of notch at the top of the wall

GUS_W = 5.0        # gusset width (at each outer end of the wall)
GUS_TOP = 11.0     # flat top depth of the gusset
GUS_FOOT = 3.0     # height of the vertical heel of the gusset above the plate
GUS_SLOPE = 45.0   # slope angle of the gusset (deg)

BOSS_D = 8.2       # front bosses (spacers) on the wall
BOSS_LEN = 4.4
BOSS_HOLE = 4.0
BOSS_X = [35.0, 68.0]
BOSS_Z = [4.7, 24.7]

SO_D = 8.2         # stand-offs on the plate
SO_H = 4.6
SO_HOLE = 4.0
STANDOFFS = [(-77.0, 226.7), (77.0, 226.7),
             (-76.8, 104.5), (77.0, 104.5),
             (77.0, 80.8), (45.3, 75.1),
             (42.2, 39.9), (10.3, 34.8)]

SLOT_W = 5.0
SLOT_R = 0.8
SLOTS = [(61.4, 51.2, 32.0), (26.6, 10.7, 32.0)]  # (x centre, y centre, length)

VIEW = {"azimuth": 45, "elevation": 26}

SLOPE = (W_BACK - W_FRONT) / 2 / TAPER_LEN   # dx/dy of the tapered edge


def half_width(y):
    """Half width of the (unblended) plate outline at distance y from front."""
    if y >= TAPER_LEN:
        return W_BACK / 2
    return W_FRONT / 2 + SLOPE * y


# ---------------- base plate ----------------
# each side edge is ONE smooth curve: straight taper, short blend, straight side
def side_curve(s):
    y1, y2 = TAPER_LEN - BLEND, TAPER_LEN + BLEND
    pts = [(s * W_FRONT / 2, 0.0), (s * half_width(y1), y1),
           (s * W_BACK / 2, y2), (s * W_BACK / 2, L)]
    tan = [(s * SLOPE, 1.0), (s * SLOPE, 1.0), (0.0, 1.0), (0.0, 1.0)]
    return pts, tan


pr, tr = side_curve(1)
pl, tl = side_curve(-1)
# the whole outline is extruded to the full wall height; everything above the
# plate that is not wall or gusset is cut away afterwards, so the plate edges,
# wall ends and gusset outer faces stay single flush faces
tall = (cq.Workplane("XY")
        .moveTo(-W_FRONT / 2, 0).lineTo(W_FRONT / 2, 0)
        .spline(pr[1:], tangents=tr, includeCurrent=True)
        .lineTo(-W_BACK / 2, L)
        .spline(list(reversed(pl))[1:],
                tangents=[(-a, -b) for (a, b) in reversed(tl)],
                includeCurrent=True)
        .close().extrude(H))

# ---------------- front wall with trapezoidal notch ----------------
XB = W_BACK / 2 + 10          # generous half width for the keep-volumes
wall_pts = [
    (-XB, T - 1), (XB, T - 1), (XB, H + 1),
    (NOTCH_TOP, H + 1), (NOTCH_TOP, H), (NOTCH_BOT, T), (-NOTCH_BOT, T),
    (-NOTCH_TOP, H), (-NOTCH_TOP, H + 1), (-XB, H + 1),
]
keep = (cq.Workplane("XZ", origin=(0, -1, 0)).polyline(wall_pts).close()
        .extrude(-(TW + 1)))

# ---------------- gussets at the outer ends ----------------
gy_end = GUS_TOP + (H - T - GUS_FOOT) / math.tan(math.radians(GUS_SLOPE))
gus_prof = [(-1, T - 1), (-1, H + 1), (GUS_TOP, H + 1), (GUS_TOP, H),
            (gy_end, T + GUS_FOOT), (gy_end, T - 1)]
for s in (-1, 1):
    g = (cq.Workplane("YZ", origin=(-XB, 0, 0))
         .polyline(gus_prof).close().extrude(2 * XB))
    yb = gy_end + 5
    strip_pts = [
        (s * (W_FRONT / 2 - GUS_W - SLOPE), -1), (s * XB, -1),
        (s * XB, yb), (s * (half_width(yb) - GUS_W), yb),
    ]
    strip = (cq.Workplane("XY", origin=(0, 0, T - 2)).polyline(strip_pts)
             .close().extrude(H + 4))
    keep = keep.union(g.intersect(strip))

cutter = (cq.Workplane("XY", origin=(0, 0, T))
          .rect(2 * XB, 2 * L, centered=True).extrude(H + 1)
          .translate((0, L / 2, 0)))
cutter = cutter.cut(keep)
body = tall.cut(cutter)

# ---------------- front bosses + through holes ----------------
def cyl(center, axis, seam_dir, r, h):
    """Cylinder with its seam line turned toward seam_dir."""
    pl = cq.Plane(origin=center, xDir=seam_dir, normal=axis)
    return cq.Workplane(pl).circle(r).extrude(h)


for bx in BOSS_X:
    for s in (-1, 1):
        for bz in BOSS_Z:
            body = body.union(cyl((s * bx, 0, bz), (0, -1, 0), (-1, 0, -0.5),
                                  BOSS_D / 2, BOSS_LEN))
for bx in BOSS_X:
    for s in (-1, 1):
        for bz in BOSS_Z:
            body = body.cut(cyl((s * bx, -(BOSS_LEN + 1), bz), (0, 1, 0),
                                (1, 0, 0.5), BOSS_HOLE / 2, BOSS_LEN + TW + 1.5))

# ---------------- stand-offs on the plate ----------------
for (sx, sy) in STANDOFFS:
    body = body.union(cyl((sx, sy, T), (0, 0, 1), (-1, 0.1, 0), SO_D / 2, SO_H))
for (sx, sy) in STANDOFFS:
    body = body.cut(cyl((sx, sy, -1), (0, 0, 1), (1, -0.1, 0),
                        SO_HOLE / 2, T + SO_H + 2))

# ---------------- slots through the plate ----------------
for (cx, cy, ln) in SLOTS:
    sl = (cq.Workplane("XY", origin=(cx, cy, -1))
          .rect(ln, SLOT_W).extrude(T + 2)
          .edges("|Z").fillet(SLOT_R))
    body = body.cut(sl)

result = body
